import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 85.0          # overall width (X)
L = 60.0          # overall length (Y)
BLK_W = 31.0      # width of each jaw block (X)
STEP_Z = 19.75    # height of lower block top / underside of front overhang
OVH = 10.6        # front overhang / bridge depth (Y)
BRIDGE_TOP = 30.1 # top of the front bridge

# jaw profile (u = distance from the outer face, z = height)
OUT_TOP = 31.75           # top of the outer face
NOTCH_PT = (3.5, 33.6)    # inner corner of the small V groove under the horn
HORN_MID = (1.25, 41.3)   # outer bulge of the horn
HORN_TIP = (3.26, 47.1)   # horn tip
CRADLE_C = (20.23, 52.63) # centre of the cradle arc
CRADLE_R = 17.89
LIP_L = (20.85, 34.72)    # foot of the lip on the cradle side
LIP_TOP_Z = 36.35
LIP_X0, LIP_X1 = 21.5, 22.6
LIP_ROUND = 0.25          # rounding of the lip crest
SHOULDER_C = (21.75, 19.57)  # centre of the inner shoulder arc
SHOULDER_R = 14.1

# front notches (vertical cylinders at the inner block edges)
NOTCH_U = 30.65    # notch centre from outer face
NOTCH_R = 7.4
NOTCH_YC = -3.68   # centre lies in front of the front face

# holes
UP_HOLE_U, UP_HOLE_Z, UP_HOLE_D, UP_HOLE_CSK = 8.5, 26.4, 4.55, 5.7
UP_HOLE_BACK_CB, UP_HOLE_BACK_CB_DEPTH = 9.0, 10.0
FR_HOLE_U, FR_HOLE_Z, FR_HOLE_D, FR_HOLE_DEPTH = 18.3, 16.1, 4.95, 15.0
FR_HOLE_CB, FR_HOLE_CB_DEPTH = 6.8, 4.0
SIDE_HOLE_Y = (20.6, 52.2)
SIDE_HOLE_Z = 8.5
SIDE_HOLE_D, SIDE_HOLE_CB, SIDE_HOLE_CB_DEPTH = 4.8, 8.7, 20.0
BK_HOLE_Z, BK_HOLE_D, BK_HOLE_DEPTH = 17.1, 7.0, 12.0
RIM_CH = 0.4  # small chamfer on the back hole rims

EPS = 0.02


def arc_pt(c, r, ang_deg):
    a = math.radians(ang_deg)
    return (c[0] + r * math.cos(a), c[1] + r * math.sin(a))


def jaw_profile_pts():
    """Helper points for the three-point arcs of the jaw outline (u, z)."""
    a_tip = math.degrees(math.atan2(HORN_TIP[1] - CRADLE_C[1], HORN_TIP[0] - CRADLE_C[0]))
    a_lip = math.degrees(math.atan2(LIP_L[1] - CRADLE_C[1], LIP_L[0] - CRADLE_C[0]))
    cradle_mid = arc_pt(CRADLE_C, CRADLE_R, 0.5 * (a_tip + a_lip))
    sh_start = (LIP_X1, SHOULDER_C[1] + math.sqrt(SHOULDER_R**2 - (LIP_X1 - SHOULDER_C[0])**2))
    sh_end = (BLK_W, BRIDGE_TOP)
    a0 = math.degrees(math.atan2(sh_start[1] - SHOULDER_C[1], sh_start[0] - SHOULDER_C[0]))
    a1 = math.degrees(math.atan2(sh_end[1] - SHOULDER_C[1], sh_end[0] - SHOULDER_C[0]))
    sh_mid = arc_pt(SHOULDER_C, SHOULDER_R, 0.5 * (a0 + a1))
    return cradle_mid, sh_start, sh_mid, sh_end


def make_jaw():
    """Left jaw (outer face at x = -W/2), full length 0..L along +Y."""
    cradle_mid, sh_start, sh_mid, sh_end = jaw_profile_pts()
    x0 = -W / 2.0

    def P(p):
        return (x0 + p[0], p[1])

    wp = (
        cq.Workplane("XZ")
        .moveTo(*P((0.0, 0.0)))
        .lineTo(*P((0.0, OUT_TOP)))
        .lineTo(*P(NOTCH_PT))
        .threePointArc(P(HORN_MID), P(HORN_TIP))
        .threePointArc(P(cradle_mid), P(LIP_L))
        .lineTo(*P((LIP_X0 - LIP_ROUND * 0.4, LIP_TOP_Z - LIP_ROUND)))
        .threePointArc(P((0.5 * (LIP_X0 + LIP_X1), LIP_TOP_Z)), P((LIP_X1, LIP_TOP_Z - LIP_ROUND)))
        .lineTo(*P(sh_start))
        .threePointArc(P(sh_mid), P(sh_end))
        .lineTo(*P((BLK_W, 0.0)))
        .close()
    )
    return wp.extrude(-L)  # XZ normal is -Y, so negative goes +Y


def bore(p, direction, dia, depth, start_out=1.0, seam=(0, 0, 1)):
    """Cylindrical tool starting start_out before point p and running depth into the part.
    The cylinder seam is turned towards `seam` (the hidden upper side of the hole)."""
    d = cq.Vector(*direction).normalized()
    base = cq.Vector(*p) - d * start_out
    sv = cq.Vector(*seam)
    sv = sv - d * sv.dot(d)
    if sv.Length < 1e-6:
        sv = cq.Vector(1, 0, 0) - d * d.x
    sv = sv.normalized()
    loc = cq.Location(cq.Plane(origin=base.toTuple(), xDir=sv.toTuple(), normal=d.toTuple()))
    cyl = cq.Solid.makeCylinder(dia / 2.0, depth + start_out, cq.Vector(0, 0, 0), cq.Vector(0, 0, 1))
    return cyl.moved(loc)


def rim_chamfer(p, direction, dia, ch):
    """Conical tool producing a 45 deg chamfer of size ch on a hole rim at p."""
    d = cq.Vector(*direction).normalized()
    r_out = dia / 2.0 + ch + 0.5
    base = cq.Vector(*p) - d * 0.5
    return cq.Solid.makeCone(r_out, 0.0, r_out, base, d)


# ---------------- main body ----------------
left = make_jaw()
right = left.mirror("YZ")

gap_half = W / 2.0 - BLK_W
bridge = cq.Workplane("XY").box(
    2 * gap_half + 2 * EPS, OVH, BRIDGE_TOP, centered=False
).translate((-gap_half - EPS, 0, 0))

body = left.union(right).union(bridge)

# clear the space under the front overhang across the whole width
under = cq.Workplane("XY").box(W + 4, OVH + EPS, STEP_Z + EPS, centered=False).translate(
    (-W / 2 - 2, -EPS, -EPS)
)
body = body.cut(under)

# vertical notches on the front face at the inner jaw edges
for s in (-1, 1):
    xc = s * (W / 2 - NOTCH_U)
    cyl = bore((xc, NOTCH_YC, STEP_Z), (0, 0, 1), 2 * NOTCH_R, 40.0)
    body = body.cut(cq.Workplane().add(cyl))

# ---------------- holes ----------------
tools = []
for s in (-1, 1):
    xu = s * (W / 2 - UP_HOLE_U)
    # upper through hole along Y: front countersink, rear counterbore
    tools.append(bore((xu, 0, UP_HOLE_Z), (0, 1, 0), UP_HOLE_D, L + 1))
    tools.append(rim_chamfer((xu, 0, UP_HOLE_Z), (0, 1, 0), UP_HOLE_D, (UP_HOLE_CSK - UP_HOLE_D) / 2))
    tools.append(bore((xu, L, UP_HOLE_Z), (0, -1, 0), UP_HOLE_BACK_CB, UP_HOLE_BACK_CB_DEPTH))
    tools.append(rim_chamfer((xu, L, UP_HOLE_Z), (0, -1, 0), UP_HOLE_BACK_CB, RIM_CH))

    # rear blind hole below it
    tools.append(bore((xu, L, BK_HOLE_Z), (0, -1, 0), BK_HOLE_D, BK_HOLE_DEPTH))
    tools.append(rim_chamfer((xu, L, BK_HOLE_Z), (0, -1, 0), BK_HOLE_D, RIM_CH))

    # counterbored blind hole in the recessed front face of the lower block
    xf = s * (W / 2 - FR_HOLE_U)
    tools.append(bore((xf, OVH, FR_HOLE_Z), (0, 1, 0), FR_HOLE_D, FR_HOLE_DEPTH))
    tools.append(bore((xf, OVH, FR_HOLE_Z), (0, 1, 0), FR_HOLE_CB, FR_HOLE_CB_DEPTH))

    # counterbored through holes across the lower block (X direction)
    for yh in SIDE_HOLE_Y:
        x_out = s * W / 2
        d = (-s, 0, 0)
        tools.append(bore((x_out, yh, SIDE_HOLE_Z), d, SIDE_HOLE_D, BLK_W + 1))
        tools.append(bore((x_out, yh, SIDE_HOLE_Z), d, SIDE_HOLE_CB, SIDE_HOLE_CB_DEPTH))

for t in tools:
    body = body.cut(cq.Workplane().add(t))

result = body
